import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Flat "cross" carrier: lower body with two side clips, upper body, a cross
# bar made of two slightly converging bars with eyelet ends, a neck, a head
# (tab + raised block with holes) and two leads (serpentine strips, one with a
# large and one with a small wave amplitude).
# Layout is drawn in a local 2D frame:  v = across the part, u = along axis
# (u = 0 at the lead tips).  The finished part lies in the XZ plane, tilted
# TILT degrees about +Y so its top leans toward +X.  Back side is +Y.
# ---------------------------------------------------------------------------
K = 0.125            # mm per layout unit
TILT = 30.0          # axis tilt from vertical
T = 6.0              # plate thickness (layout units)

# lower body (trapezoid, widening upward)
LB_U0, LB_U1 = 360.0, 485.0
LB_BOT = (-24.0, 25.0)
LB_TOP = (-28.0, 31.0)

# side clips (ears) + band on the back
LCLIP = (-44.0, -20.0, 478.0, 515.0)   # v0, v1, u0, u1
RCLIP = (24.0, 50.0, 483.0, 536.0)
CLIP_R = 6.0
CLIP_BAND_H = 2.5                  # back side
CLIP_BAND_F = 0.5                  # front side
CLIP_HOLE_D = 3.5

# upper body
UB_V = (-31.0, 34.0)
UB_V1_TOP = 40.0               # right edge widens slightly toward the head
UB_U0, UB_U1 = 480.0, 665.0
UB_RIGHT_TOP = 716.0           # right-hand strip of upper body reaches higher
NOTCH = (27.0, 715.0, 737.0)   # inner v, u0, u1 of U-notch under head block

COVER = (485.0, 664.0, 24.0)   # u0, u1, right edge v of thin front layer
COVER_T = 0.8

# neck
NK_V = (-16.0, 30.0)             # left edge leans in to NK_V_TOP at the head
NK_V_TOP = -12.0
NK_U0, NK_U1 = 655.0, 745.0
NK_FILLET = 16.0

# head: tab (left) and raised block (right)
TAB = (-34.0, -12.0, 726.0, 831.0)
TAB_R = 5.0
TAB_HOLE = (-27.0, 823.0, 8.0)          # v, u, diameter
BLK = (-13.0, 43.0, 738.0, 861.0)
BLK_R = 8.0
BLK_RAISE = 1.0                         # block stands proud of front face
BLK_HOLES = [(0.5, 850.0), (15.5, 850.0), (31.0, 850.0)]
BLK_HOLE_D = 8.0

# cross bar: two bars (A upper/back, B lower/front) converging to the right
BAR_A = ((-120.0, 631.0), (139.0, 628.0), 26.0)  # left centre, right centre, width
BAR_B = ((-108.0, 609.0), (143.0, 622.0), 24.0)
BAR_HOLE_D = 8.5
BAR_SHIFT_A = 0.4                  # bars sit this much toward the front
BAR_SHIFT_B = 1.0
BAR_BACK = 0.5                     # bars also stand proud of the back face

# pins (rivets) through the cross bar, protruding on the back
PIN_H = 7.5
PIN_HEAD = 0.6
PINS = [((-106.0, 622.0), 12.0),
        ((89.0, 620.0), 9.0), ((109.0, 621.0), 11.0),
        ((126.0, 622.0), 11.0), ((137.0, 637.0), 7.0)]

# leads
LEAD_W = 12.5
LEAD_T = 5.0
WAVE_AMP = 2.4
WAVE_PERIOD = 28.0
R_LEAD_TOP = (8.5, 372.0)        # (v, u) where serpentine strip enters body
R_LEAD_TIP = (12.8, 13.0)
R_LEAD_STRAIGHT = 55.0
L_LEAD_TOP = (-7.0, 372.0)
L_LEAD_TIP = (-12.8, -13.0)
L_LEAD_STRAIGHT = 45.0
L_WAVE_AMP = 1.4                 # low-amplitude serpentine (braided lead)
L_WAVE_PERIOD = 25.0
L_LEAD_W = 12.5
L_LEAD_T = 4.5


# ----------------------------------------------------------------- helpers
def wp_at(y_front):
    """XZ workplane whose plane sits at Y = y_front (extrude(-d) goes +Y)."""
    return cq.Workplane("XZ").workplane(offset=-y_front)


def plate(pts, t=T, y0=-T / 2):
    return wp_at(y0).polyline(pts).close().extrude(-t)


def rrect(v0, v1, u0, u1, r, t=T, y0=-T / 2):
    return (wp_at(y0).center((v0 + v1) / 2, (u0 + u1) / 2)
            .sketch().rect(v1 - v0, u1 - u0).vertices().fillet(r).finalize()
            .extrude(-t))


def slot_bar(p0, p1, w, t=T, y0=-T / 2):
    (v0, u0), (v1, u1) = p0, p1
    length = math.hypot(v1 - v0, u1 - u0)
    ang = math.degrees(math.atan2(u1 - u0, v1 - v0))
    return (wp_at(y0).center((v0 + v1) / 2, (u0 + u1) / 2)
            .slot2D(length + w, w, ang).extrude(-t))


def cut_holes(body, pts, d):
    tool = wp_at(-50).pushPoints(pts).circle(d / 2).extrude(-100)
    return body.cut(tool)


# ----------------------------------------------------------------- body
body = plate([(LB_BOT[0], LB_U0), (LB_BOT[1], LB_U0),
              (LB_TOP[1], LB_U1), (LB_TOP[0], LB_U1)])
body = body.union(plate([(UB_V[0], UB_U0), (UB_V[1], UB_U0),
                         (UB_V1_TOP, UB_RIGHT_TOP), (NOTCH[0] - 1, UB_RIGHT_TOP),
                         (NOTCH[0] - 1, UB_U1), (UB_V[0], UB_U1)]))
# neck with concave fillets into the head tab
neck = plate([(NK_V[0], NK_U0), (NK_V[1], NK_U0), (NK_V[1], NK_U1),
               (NK_V_TOP, NK_U1)])
body = body.union(neck)

# thin front cover layer on the upper body
body = body.union(plate([(UB_V[0], COVER[0]), (COVER[2], COVER[0]),
                         (COVER[2], COVER[1]), (UB_V[0], COVER[1])],
                        t=COVER_T, y0=-T / 2 - COVER_T))

# side clips
body = body.union(rrect(*LCLIP, CLIP_R)).union(rrect(*RCLIP, CLIP_R))

# head
body = body.union(rrect(*TAB, TAB_R))
body = body.union(rrect(*BLK, BLK_R, t=T + BLK_RAISE, y0=-T / 2 - BLK_RAISE))

# concave fillet between neck and tab (left side)
fil = (wp_at(-T / 2).center(NK_V_TOP - NK_FILLET, TAB[2] - NK_FILLET)
       .rect(NK_FILLET + 1.0, NK_FILLET, centered=False).extrude(-T))
fil_cut = (wp_at(-T / 2 - 1).center(NK_V_TOP - NK_FILLET, TAB[2] - NK_FILLET)
           .circle(NK_FILLET).extrude(-T - 2))
body = body.union(fil.cut(fil_cut))

# cross bar
body = body.union(slot_bar(*BAR_A, t=T + BAR_SHIFT_A + BAR_BACK,
                           y0=-T / 2 - BAR_SHIFT_A))
body = body.union(slot_bar(*BAR_B, t=T + BAR_SHIFT_B + BAR_BACK - 0.3,
                           y0=-T / 2 - BAR_SHIFT_B))

# U-notch between head block and upper body (right side)
nw = NOTCH[2] - NOTCH[1]
notch = (wp_at(-50).center(NOTCH[0] + (80.0 + nw) / 2, (NOTCH[1] + NOTCH[2]) / 2)
         .slot2D(80.0 + nw, nw, 0).extrude(-100))
body = body.cut(notch)

# back-side bands of the clips
for c in (LCLIP, RCLIP):
    band = rrect(LCLIP[0] + 2, RCLIP[1] - 2, c[2] + 4, c[3] - 4, 3.0,
                 t=CLIP_BAND_H, y0=T / 2)
    body = body.union(band)
    band = rrect(LCLIP[0] + 2, RCLIP[1] - 2, c[2] + 4, c[3] - 4, 3.0,
                 t=CLIP_BAND_F, y0=-T / 2 - CLIP_BAND_F)
    body = body.union(band)

# pins / rivets
for (v, u), d in PINS:
    y_front = -T / 2 - BAR_SHIFT_B - PIN_HEAD
    pin = (wp_at(y_front).center(v, u).circle(d / 2)
           .extrude(-(T / 2 + PIN_H - y_front)))
    body = body.union(pin)

# holes
body = cut_holes(body, [(TAB_HOLE[0], TAB_HOLE[1])], TAB_HOLE[2])
body = cut_holes(body, BLK_HOLES, BLK_HOLE_D)
body = cut_holes(body, [BAR_A[0], BAR_B[0], BAR_B[1]], BAR_HOLE_D)
body = cut_holes(body, [(LCLIP[0] + 8, LCLIP[2] + 6), (LCLIP[0] + 16, LCLIP[2] + 8),
                        (RCLIP[1] - 8, RCLIP[2] + 6), (RCLIP[1] - 16, RCLIP[2] + 8)],
                 CLIP_HOLE_D)


# ----------------------------------------------------------------- leads
def wavy_strip(top, tip, straight, amp, period, w, t, lateral_in_plane=True):
    """Strip from tip to top: straight end section, then a sinuous section.
    The wave runs in-plane (serpentine) or out of plane along Y (corrugated).
    The wave outline (two offset sine edges + end lines) is drawn in the
    plane of the wave and extruded across the strip."""
    (vt, ut), (vb, ub) = top, tip
    L = math.hypot(vt - vb, ut - ub)
    axis = cq.Vector((vt - vb) / L, 0, (ut - ub) / L)
    inplane_n = cq.Vector(axis.z, 0, -axis.x)
    if lateral_in_plane:
        lat, ext, thick, width = inplane_n, cq.Vector(0, 1, 0), t, w
    else:
        lat, ext, thick, width = cq.Vector(0, 1, 0), inplane_n, w, t
    base = cq.Vector(vb, 0, ub)
    wave_len = L - straight
    n_half = max(2, int(round(wave_len / (period / 2))))
    k = math.pi * n_half / wave_len

    def centre(s):
        if s <= straight:
            return -amp, 0.0
        x = s - straight
        return -amp * math.cos(k * x), amp * k * math.sin(k * x)

    def P(s, side):
        off, slope = centre(s)
        ln = math.hypot(1.0, slope)
        a = s - side * slope / ln * width / 2
        b = off + side / ln * width / 2
        return base + axis * a + lat * b

    samples = [straight + wave_len * i / (4 * n_half)
               for i in range(4 * n_half + 1)]
    sides = [cq.Edge.makeSpline([P(s, sd) for s in samples]) for sd in (1, -1)]
    r0, l0 = P(0, 1), P(0, -1)
    wire = cq.Wire.assembleEdges([
        cq.Edge.makeLine(l0, r0),
        cq.Edge.makeLine(r0, sides[0].startPoint()),
        sides[0],
        cq.Edge.makeLine(sides[0].endPoint(), sides[1].endPoint()),
        sides[1],
        cq.Edge.makeLine(l0, sides[1].startPoint())])
    face = cq.Face.makeFromWires(wire)
    solid = cq.Solid.extrudeLinear(face, ext * thick)
    return cq.Workplane("XY").add(solid.translate(ext * (-thick / 2)))


rlead = wavy_strip(R_LEAD_TOP, R_LEAD_TIP, R_LEAD_STRAIGHT, WAVE_AMP,
                   WAVE_PERIOD, LEAD_W, LEAD_T, lateral_in_plane=True)
llead = wavy_strip(L_LEAD_TOP, L_LEAD_TIP, L_LEAD_STRAIGHT, L_WAVE_AMP,
                   L_WAVE_PERIOD, L_LEAD_W, L_LEAD_T, lateral_in_plane=True)

part = body.union(rlead).union(llead)

# ----------------------------------------------------------------- place
shape = part.val().scale(K)
shape = shape.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 1, 0), TILT)
result = cq.Workplane("XY").add(shape)

VIEW = {"azimuth": 45, "elevation": 26}
